import math
import cadquery as cq

# =====================================================================
#  Tilted display bezel: rounded-rectangle flange leaning back 10 deg,
#  tapered rectangular tube behind it ending in a vertical back plane,
#  four screw lugs on the back plane, catch ribs on the flange back.
#  X = width, Z = height, Y = depth (front of the bezel faces -Y).
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
TILT = 10.0            # flange tilt about X (top leans back towards +Y)
FL_W = 120.0           # flange outer width  (X)
FL_H = 115.8           # flange outer height (Z)
FL_T = 4.7             # flange thickness (normal to its faces)
FL_R = 15.0            # flange outer corner radius
CH_OUT = 2.5           # chamfer on the front outer edge
CH_IN = 2.5            # chamfer on the front opening edge
FL_Y0 = -5.94          # Y of the flange front face at Z = 0

Y_BACK = 16.15         # back plane of the tube (lug faces)
TUBE_HW = 48.5         # tube outer half width
WALL = 2.5             # tube wall thickness
TOP_OUT = 43.8         # tube outer top at the back plane
BOT_OUT = -39.6        # tube outer bottom at the back plane
DRAFT = 9.0            # top / bottom wall taper (deg): opening narrows to the back
R_OUT = 8.3            # tube outer corner radius
R_IN = 5.8             # tube inner corner radius

LUG_X_TOP = 35.0       # top lug centre offset in X
LUG_X_BOT = 33.5       # bottom lug centre offset in X
LUG_W = 7.4            # lug width
LUG_H = 6.8            # lug height above / below the tube wall
LUG_FLAT = 2.5         # lug depth at its tip
LUG_BASE = 7.5         # lug depth where it meets the tube wall
LUG_HOLE = 3.4         # lug hole diameter

RIB_TB_HALF = 23.0     # half length of the top / bottom catch ribs
RIB_TOP_Z = 56.0       # flat (upper) face of the top catch rib
RIB_TOP_LEN = 5.2      # footprint height of the top rib on the flange
RIB_TOP_Y = 12.0       # back face of the top rib
RIB_TOP_BACK = 1.5     # height of the top rib back face
RIB_BOT_Z = -55.7      # flat (lower) face of the bottom catch rib
RIB_BOT_LEN = 6.2      # footprint height of the bottom rib on the flange
RIB_BOT_Y = -7.4       # back face of the bottom rib
RIB_BOT_BACK = 3.2     # height of the bottom rib back face

HOOK_XC = 54.3         # side hook: inner face X
HOOK_XA = 55.5         # side hook: root of the undercut on the flange
HOOK_XB = 58.0         # side hook: outer face X
HOOK_D1 = 3.0          # side hook: depth where the undercut ends (barb edge)
HOOK_RAMP = 0.9        # side hook: inward run of the lead-in ramp behind the barb
HOOK_D = 4.6           # side hook: total stand-off from the flange back
HOOK_HALF = 20.8       # side hook half length (along the flange)
HOOK_Z0 = 0.6          # side hook centre height

# ---------------- derived ----------------
t = math.radians(TILT)
TT = math.tan(t)
FL_TY = FL_T / math.cos(t)          # flange thickness measured along Y
FL_YB0 = FL_Y0 + FL_TY              # Y of the flange back face at Z = 0
N_FRONT = cq.Vector(0, -math.cos(t), math.sin(t))   # outward normal of the front face


def y_back_face(z):
    return FL_YB0 + z * TT


def rrect_wire(y, hw, z0, z1, r):
    """rounded rectangle wire in the plane Y=y, X in [-hw, hw], Z in [z0, z1]"""
    pts = [
        cq.Vector(-hw, y, z0),
        cq.Vector(hw, y, z0),
        cq.Vector(hw, y, z1),
        cq.Vector(-hw, y, z1),
    ]
    w = cq.Wire.makePolygon(pts, close=True)
    return w.fillet2D(r, w.Vertices())


def loft_box(y0, y1, hw, zt0, zb0, zt1, zb1, r):
    """straight-sided (ruled) loft between two rounded rectangles"""
    w0 = rrect_wire(y0, hw, zb0, zt0, r)
    w1 = rrect_wire(y1, hw, zb1, zt1, r)
    return cq.Solid.makeLoft([w0, w1], True)


def slab(y_at_z0, thick_y, big=200.0):
    """half-space slab bounded by two planes tilted like the flange"""
    yz = [
        (y_at_z0 - big * TT, -big),
        (y_at_z0 + thick_y - big * TT, -big),
        (y_at_z0 + thick_y + big * TT, big),
        (y_at_z0 + big * TT, big),
    ]
    return (cq.Workplane("YZ", origin=(-big, 0, 0)).polyline(yz).close()
            .extrude(2 * big).val())


def to_flange_frame(shape):
    """flange frame (x, thickness y from the front face, z along the face) -> world"""
    return shape.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -TILT).translate(
        cq.Vector(0, FL_Y0, 0))


# ---------------- flange ----------------
# rounded-rectangle outline extruded along Y, trimmed by the two tilted faces:
# sides / top / bottom stay square to the world, front and back lean back.
outline = (
    cq.Workplane("XZ", origin=(0, 40, 0))
    .sketch().rect(FL_W, FL_H).vertices().fillet(FL_R).finalize()
    .extrude(80)               # XZ normal is -Y: runs from Y=40 to Y=-40
)
flange = outline.intersect(cq.Workplane().add(slab(FL_Y0, FL_TY)))

# ---------------- tube (tapered) ----------------
tg = math.tan(math.radians(DRAFT))
y_start = -30.0
L = Y_BACK - y_start
tube_out = loft_box(y_start, Y_BACK, TUBE_HW,
                    TOP_OUT + L * tg, BOT_OUT - L * tg, TOP_OUT, BOT_OUT, R_OUT)
# keep only the part behind the flange front face
tube_out = cq.Workplane().add(tube_out).intersect(
    cq.Workplane().add(slab(FL_Y0, 100.0)))

body = flange.union(tube_out)


# ---------------- screw lugs on the back plane ----------------
def lug(xc, top=True):
    s = 1 if top else -1
    z_wall = TOP_OUT if top else BOT_OUT
    r = LUG_W / 2
    z_tip = z_wall + s * LUG_H
    zc = z_tip - s * r
    z_root = z_wall - s * 2.0
    # outline seen from the back (round-ended tab), extruded forward from the back plane
    tab = (
        cq.Workplane("XZ", origin=(0, Y_BACK, 0))
        .moveTo(xc - r, z_root).lineTo(xc - r, zc)
        .threePointArc((xc, z_tip), (xc + r, zc))
        .lineTo(xc + r, z_root).close()
        .extrude(LUG_BASE + 3)
    )
    # side outline: short flat at the tip, sloped gusset down to the wall
    side = (
        cq.Workplane("YZ", origin=(xc - r - 1, 0, 0))
        .polyline([
            (Y_BACK, z_root),
            (Y_BACK, z_tip + s),
            (Y_BACK - LUG_FLAT, z_tip + s),
            (Y_BACK - LUG_FLAT, z_tip),
            (Y_BACK - LUG_BASE, z_wall),
            (Y_BACK - LUG_BASE - 3, z_wall - s * 0.5),
            (Y_BACK - LUG_BASE - 3, z_root),
        ]).close()
        .extrude(LUG_W + 2)
    )
    hole = (cq.Workplane("XZ", origin=(0, Y_BACK + 1, 0)).center(xc, zc)
            .circle(LUG_HOLE / 2).extrude(LUG_BASE + 1))
    return tab.intersect(side), hole


holes = []
for xc, top in ((-LUG_X_TOP, True), (LUG_X_TOP, True), (-LUG_X_BOT, False), (LUG_X_BOT, False)):
    lb, h = lug(xc, top)
    body = body.union(lb)
    holes.append(h)


# ---------------- catch ribs on the flange back ----------------
def tb_rib(z_flat, z_end, y_tip, x_half, back_h):
    """wedge rib: flat face outwards, back face, ramp down to the flange"""
    yf = y_back_face(z_flat)
    ye = y_back_face(z_end)
    s_ = 1 if z_flat > z_end else -1
    pts = [
        (yf - 1.5, z_flat),
        (y_tip, z_flat),
        (y_tip, z_flat - s_ * back_h),
        (ye, z_end),
        (ye - 1.5, z_end),
    ]
    return (cq.Workplane("YZ", origin=(-x_half, 0, 0)).polyline(pts).close()
            .extrude(2 * x_half))


body = body.union(tb_rib(RIB_TOP_Z, RIB_TOP_Z - RIB_TOP_LEN, RIB_TOP_Y, RIB_TB_HALF, RIB_TOP_BACK))
body = body.union(tb_rib(RIB_BOT_Z, RIB_BOT_Z + RIB_BOT_LEN, RIB_BOT_Y, RIB_TB_HALF, RIB_BOT_BACK))

# side hooks, built in the flange frame so they follow the tilted back face:
# narrow root on the flange, barb overhanging outwards (undercut), lead-in ramp behind it
for sx in (1, -1):
    pts = [
        (sx * HOOK_XC, FL_T - 1.0),
        (sx * HOOK_XC, FL_T + HOOK_D),
        (sx * (HOOK_XB - HOOK_RAMP), FL_T + HOOK_D),
        (sx * HOOK_XB, FL_T + HOOK_D1),
        (sx * HOOK_XA, FL_T),
        (sx * HOOK_XA, FL_T - 1.0),
    ]
    z0 = (HOOK_Z0 + FL_T * math.sin(t)) / math.cos(t)
    hook = (cq.Workplane("XY", origin=(0, 0, z0 - HOOK_HALF)).polyline(pts).close()
            .extrude(2 * HOOK_HALF))
    body = body.union(cq.Workplane().add(to_flange_frame(hook.val())))

# ---------------- through opening (tapered cavity) ----------------
y0 = y_start - 10
top_in = TOP_OUT - WALL
bot_in = BOT_OUT + WALL
cav = loft_box(y0, Y_BACK + 1, TUBE_HW - WALL,
               top_in + (Y_BACK - y0) * tg, bot_in - (Y_BACK - y0) * tg,
               top_in - 1 * tg, bot_in + 1 * tg, R_IN)
body = body.cut(cq.Workplane().add(cav))

for h in holes:
    body = body.cut(h)

# ---------------- front edge chamfers ----------------
front_faces = [f for f in body.faces().vals()
               if f.geomType() == "PLANE" and f.normalAt().dot(N_FRONT) > 0.999]
front = max(front_faces, key=lambda f: f.Area())
outer_edges = front.outerWire().Edges()
body = body.newObject(outer_edges).chamfer(CH_OUT)

front_faces = [f for f in body.faces().vals()
               if f.geomType() == "PLANE" and f.normalAt().dot(N_FRONT) > 0.999]
front = max(front_faces, key=lambda f: f.Area())
inner_edges = [e for w in front.innerWires() for e in w.Edges()]
body = body.newObject(inner_edges).chamfer(CH_IN)

result = body
